import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_L = 100.0        # square sheet side
PLATE_T = 0.05         # sheet thickness (thin foil-like sheet)

# small wire hook standing on the sheet, just off its centre
U = PLATE_L / 237.0    # layout unit for the hook (~0.42 mm)
HOOK_ROOT = (2.75 * U, -6.25 * U)     # where the wire is set into the sheet
HOOK_DIR_DEG = -64.0                  # plan direction in which the hook leans and curls
WIRE_D = 0.45          # wire size (across flats of its hexagonal section)
HEX_ROT = 30.0         # rotation of the hexagonal section about the wire axis (deg)

# slot in the sheet that takes the wire end (longer across the hook plane)
SLOT_LEN = 1.05
SLOT_WID = 0.40

# small low dome (weld / glue spot) on the sheet just behind the hook
DOME_POS = (1.40 * U, -3.50 * U)
DOME_R = 0.35          # base radius
DOME_H = 0.09          # height

# wire centre-line in its own vertical plane:
# (distance from the root along HOOK_DIR, height above the sheet bottom), in U
HOOK_CL = [
    (0.00, 0.00),    # wire end, flush with the underside of the sheet
    (0.25, 0.95),    # stem rising
    (1.20, 2.45),    # stem leaning forward
    (2.50, 3.55),
    (3.90, 3.85),    # crown
    (5.10, 3.45),
    (5.65, 2.70),    # tip curling back down
]

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- hook frame ----------------
d = cq.Vector(math.cos(math.radians(HOOK_DIR_DEG)), math.sin(math.radians(HOOK_DIR_DEG)), 0.0)
n = cq.Vector(0, 0, 1).cross(d).normalized()          # normal of the hook plane
o = cq.Vector(HOOK_ROOT[0], HOOK_ROOT[1], 0.0)

# ---------------- sheet with the slot for the hook ----------------
plate = cq.Workplane("XY").box(PLATE_L, PLATE_L, PLATE_T, centered=(True, True, False))
slot = (
    cq.Workplane("XY")
    .center(HOOK_ROOT[0], HOOK_ROOT[1])
    .slot2D(SLOT_LEN, SLOT_WID, HOOK_DIR_DEG + 90.0)
    .extrude(PLATE_T * 3)
    .translate((0, 0, -PLATE_T))
)
plate = plate.cut(slot)

# ---------------- low dome on the sheet ----------------
sph_r = (DOME_R ** 2 + DOME_H ** 2) / (2.0 * DOME_H)
dome = (
    cq.Workplane("XY")
    .sphere(sph_r)
    .translate((DOME_POS[0], DOME_POS[1], PLATE_T + DOME_H - sph_r))
    .intersect(
        cq.Workplane("XY")
        .center(DOME_POS[0], DOME_POS[1])
        .circle(DOME_R * 1.05)
        .extrude(DOME_H + PLATE_T)
    )
)

# ---------------- hook: hexagonal wire swept along a planar centre-line ----------------
pts = [o + d * (s * U) + cq.Vector(0, 0, z * U) for (s, z) in HOOK_CL]
path_edge = cq.Edge.makeSpline(pts, tangents=[cq.Vector(0, 0, 1), (pts[-1] - pts[-2]).normalized()])
path = cq.Wire.assembleEdges([path_edge])

c30, s30 = math.cos(math.radians(HEX_ROT)), math.sin(math.radians(HEX_ROT))
x_sec = n * c30 + d * s30                              # section x-axis, turned about the wire axis
prof_plane = cq.Plane(origin=pts[0], xDir=x_sec, normal=cq.Vector(0, 0, 1))
hook = (
    cq.Workplane(prof_plane)
    .polygon(6, WIRE_D / math.cos(math.pi / 6))
    .sweep(cq.Workplane().add(path), isFrenet=False)
)

result = plate.union(dome).union(hook)
